import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_FLANGE = 30.0        # flange outer radius
W = 26.9               # overall axial width (flange face to flange face)
T_FLANGE = 0.85        # flange thickness at tooth tip (base)
T_FLANGE_TOP = 0.6     # flange thickness at outer rim (drafted inner face)
R_TIP = 27.3           # tooth tip radius
N_TEETH = 16           # number of teeth
TOOTH_PHASE = 0.0      # groove angular offset, in pitches, from +Y
GROOVE_DEPTH = 3.2     # tooth groove depth
GROOVE_TOP_W = 7.5     # groove width at tip circle
GROOVE_BOT_W = 3.8     # groove width at root
TOOTH_FIL = 0.8        # rounding of tooth tip / root corners
R_IN = 22.35           # rim inner (recess) radius
CH_IN = 0.7            # chamfer on flange inner edge
R_HUB = 7.85           # hub outer radius
HUB_CH = 0.55          # chamfer on hub end outer edge
R_BORE = 4.45          # bore radius
R_CBORE = 5.2          # counterbore radius
CBORE_CH = 0.45        # chamfer at counterbore mouth
CBORE_DEPTH = 2.0      # counterbore depth
HUB_RECESS = 0.3       # hub end face set back from flange face
T_WEB = 3.4            # spoke axial thickness
N_SPOKES = 3
SPOKE_W = 3.4          # spoke width
SPOKE_FIL = 3.0        # blend radius spoke -> rim
SPOKE_FIL_HUB = 4.0    # blend radius spoke -> hub

SEAM_UP = 90.0         # revolve seams placed at +Z (hidden in the default view)
SEAM_DN = -90.0        # revolve seams placed at -Z

VIEW = {"azimuth": 45, "elevation": 26}

XF = W / 2.0
XH = XF - HUB_RECESS
TW = T_WEB / 2.0
R_ROOT = R_TIP - GROOVE_DEPTH


def yz(x0):
    """Workplane in the YZ plane at axial position x0 (normal +X)."""
    return cq.Workplane("YZ", origin=(x0, 0, 0))


def rot2(p, a):
    c, s = math.cos(a), math.sin(a)
    return (p[0] * c - p[1] * s, p[0] * s + p[1] * c)


# ---------------- toothed rim (2D profile with rounded corners) ----------------
ext = 1.0
slope = (GROOVE_TOP_W - GROOVE_BOT_W) / 2.0 / GROOVE_DEPTH
groove_pts = [
    (-GROOVE_BOT_W / 2, R_ROOT),
    (GROOVE_BOT_W / 2, R_ROOT),
    (GROOVE_TOP_W / 2 + slope * ext, R_TIP + ext),
    (-GROOVE_TOP_W / 2 - slope * ext, R_TIP + ext),
]
pitch = 2 * math.pi / N_TEETH
sk = cq.Sketch().circle(R_TIP)
for i in range(N_TEETH):
    # sketch x = world Y, sketch y = world Z; groove centre measured from +Z here
    a = pitch * (i + TOOTH_PHASE) - math.pi / 2
    rp = [rot2(p, a) for p in groove_pts]
    sk = sk.polygon(rp + [rp[0]], mode="s")
sk = sk.reset().vertices().fillet(TOOTH_FIL).reset().circle(R_IN - 0.5, mode="s")
teeth = yz(-XF).placeSketch(sk).extrude(W)

# flanges: flat outer face, drafted (conical) inner face
draft = (T_FLANGE - T_FLANGE_TOP) / (R_FLANGE - R_TIP)
t_root = T_FLANGE + draft * (R_TIP - R_ROOT + 0.5)
fl_pts = [
    (-XF, R_IN - 0.5),
    (-XF, R_FLANGE),
    (-XF + T_FLANGE_TOP, R_FLANGE),
    (-XF + t_root, R_ROOT - 0.5),
    (-XF + t_root, R_IN - 0.5),
]
flange = (
    cq.Workplane("XY").polyline(fl_pts).close().revolve(360, (0, 0, 0), (1, 0, 0))
    .rotate((0, 0, 0), (1, 0, 0), SEAM_DN)
)
flange2 = flange.mirror("YZ")
rim = teeth.union(flange).union(flange2)

# inner recess with chamfered edges (revolved cutter, axis = X)
rec_pts = [
    (-XF - 1, 0),
    (XF + 1, 0),
    (XF + 1, R_IN + CH_IN + 1),
    (XF - CH_IN, R_IN),
    (-XF + CH_IN, R_IN),
    (-XF - 1, R_IN + CH_IN + 1),
]
recess = (
    cq.Workplane("XY").polyline(rec_pts).close().revolve(360, (0, 0, 0), (1, 0, 0))
    .rotate((0, 0, 0), (1, 0, 0), SEAM_UP)
)
rim = rim.cut(recess)

# ---------------- hub ----------------
hub_pts = [
    (-XH, 0),
    (XH, 0),
    (XH, R_HUB - HUB_CH),
    (XH - HUB_CH, R_HUB),
    (-XH + HUB_CH, R_HUB),
    (-XH, R_HUB - HUB_CH),
]
hub = (
    cq.Workplane("XY").polyline(hub_pts).close().revolve(360, (0, 0, 0), (1, 0, 0))
    .rotate((0, 0, 0), (1, 0, 0), SEAM_DN)
)

# ---------------- three spokes with rolling-ball blends to hub and rim ----------------
body = rim.union(hub)
for i in range(N_SPOKES):
    ang = 90 + 360.0 / N_SPOKES * i
    spoke = (
        cq.Workplane("XY")
        .box(T_WEB, R_IN - R_HUB + 2.0, SPOKE_W)
        .translate((0, (R_IN + R_HUB) / 2.0, 0))
        .rotate((0, 0, 0), (1, 0, 0), ang)
    )
    body = body.union(spoke)


def _junction_edges(shape, r, tol=1e-3):
    """Edges where the spokes meet the cylinder of radius r (within the web)."""
    out = []
    for e in shape.Edges():
        ok = True
        for t in (0.0, 0.5, 1.0):
            p = e.positionAt(t)
            if abs(math.hypot(p.y, p.z) - r) > tol or abs(p.x) > TW + tol:
                ok = False
                break
        if ok:
            out.append(e)
    return out


sol = body.val()
sol = sol.fillet(SPOKE_FIL_HUB, _junction_edges(sol, R_HUB))
sol = sol.fillet(SPOKE_FIL, _junction_edges(sol, R_IN))
body = cq.Workplane("XY").add(sol)

# ---------------- bore, counterbores ----------------
bore_pts = [
    (-XH - 1, 0),
    (XH + 1, 0),
    (XH + 1, R_CBORE + CBORE_CH + 1),
    (XH, R_CBORE + CBORE_CH),
    (XH - CBORE_CH, R_CBORE),
    (XH - CBORE_DEPTH, R_CBORE),
    (XH - CBORE_DEPTH, R_BORE),
    (-XH + CBORE_DEPTH, R_BORE),
    (-XH + CBORE_DEPTH, R_CBORE),
    (-XH + CBORE_CH, R_CBORE),
    (-XH, R_CBORE + CBORE_CH),
    (-XH - 1, R_CBORE + CBORE_CH + 1),
]
bore = (
    cq.Workplane("XY").polyline(bore_pts).close().revolve(360, (0, 0, 0), (1, 0, 0))
    .rotate((0, 0, 0), (1, 0, 0), SEAM_UP)
)
body = body.cut(bore)

result = body
